import math
import cadquery as cq

# Driving dimensions (mm)
D_SMALL = 200.0      # outer diameter of the cylindrical spigot
D_LARGE = 290.0      # outer diameter of the cone mouth
L_CYL = 49.0         # length of the cylindrical spigot
L_CONE = 78.5        # axial length of the conical section
T = 5.4              # sheet wall thickness
SEAM_ANGLE = 90.0    # rotation of the revolve seam about the axis (cosmetic)

R1 = D_SMALL / 2.0
R2 = D_LARGE / 2.0

# inward normal of the cone wall (in r, y coordinates)
dr, dy = R2 - R1, L_CONE
ln = math.hypot(dr, dy)
nr, ny = -dy / ln, dr / ln

# inner cone line: p(s) = (R1 + T*nr, L_CYL + T*ny) + s*(dr, dy)
p0r, p0y = R1 + T * nr, L_CYL + T * ny
# intersection with inner cylinder r = R1 - T
s_a = ((R1 - T) - p0r) / dr
ia = (R1 - T, p0y + s_a * dy)
# intersection with end plane y = L_CYL + L_CONE
s_b = ((L_CYL + L_CONE) - p0y) / dy
ib = (p0r + s_b * dr, L_CYL + L_CONE)

pts = [
    (R1 - T, 0.0),
    (R1, 0.0),
    (R1, L_CYL),
    (R2, L_CYL + L_CONE),
    ib,
    ia,
]

# profile drawn in the XY plane (x = radius, y = axial) and revolved about Y
result = (
    cq.Workplane("XY")
    .polyline(pts)
    .close()
    .revolve(360.0, (0, 0, 0), (0, 1, 0))
)
# put the revolve seam underneath, centre the part along its axis, small spigot toward -Y
result = result.rotate((0, 0, 0), (0, 1, 0), SEAM_ANGLE)
result = result.translate((0, -(L_CYL + L_CONE) / 2.0, 0))

VIEW = {"azimuth": 45, "elevation": 26}
